import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Rotary encoder, shaft along +Y, PCB pins bent toward -Y.
BODY_W = 12.0          # X
BODY_H = 11.6          # Z
BODY_D = 4.0           # Y depth of the square housing
BODY_R_CORNER = 0.55   # rounding of the edges running along Y
BODY_R_EDGE = 0.12     # rounding of the front / back face borders

FLANGE_D = 8.3         # round boss on the back face
FLANGE_T = 1.92
KEY_W = 2.0            # key blocks at 12 and 6 o'clock on the boss
KEY_TOP_GAP = 0.12

BUSH_D = 6.5           # bushing (thread not modelled)
BUSH_L = 7.1
NECK_D = 5.2
NECK_L = 0.5
SHAFT_D = 6.0
SHAFT_L = 12.0
FLAT_START = 2.15      # round length before the D-flat
FLAT_H = 1.52          # flat distance from shaft axis
SHAFT_END_R = 0.35

PIN_PITCH = 2.5
PIN_W = 1.0            # strip width (Z)
PIN_T = 0.22           # strip thickness
PIN_Y_OFF = 1.2        # distance from front face to back of the pin strip
PIN_OUT_L = 1.62       # -X pins reach out of the housing
PIN_OUT_R = 1.14       # +X pins reach out of the housing
PIN_LEN = 4.1          # pin reach beyond the front face
PIN_CH = 0.3

TAB_W = 2.05           # mounting tabs on top / bottom
TAB_T = 0.2
TAB_REACH = 4.0        # beyond the front face

SIDE_TAB_T = 0.36      # thin ground tab on -X side at the back
SIDE_TAB_H = 2.0
SIDE_TAB_IN = 0.44
SIDE_TAB_OUT = 2.6

Y_FRONT = -BODY_D
Y_BACK = 0.0


def ybox(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def ycyl(d, y0, y1):
    # cylinder along +Y; seam turned toward the (-X,-Z) diagonal (out of sight)
    c = cq.Solid.makeCylinder(d / 2.0, y1 - y0, cq.Vector(0, y0, 0), cq.Vector(0, 1, 0))
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -135)
    return cq.Workplane("XY").add(c)


def thick_polyline(pts, t):
    """Closed outline of a polyline of thickness t (mitered joins)."""
    n = len(pts)
    normals = []
    for i in range(n - 1):
        (x0, y0), (x1, y1) = pts[i], pts[i + 1]
        dx, dy = x1 - x0, y1 - y0
        L = math.hypot(dx, dy)
        normals.append((-dy / L, dx / L))
    left, right = [], []
    for i, (x, y) in enumerate(pts):
        if i == 0:
            nx, ny = normals[0]
        elif i == n - 1:
            nx, ny = normals[-1]
        else:
            a, b = normals[i - 1], normals[i]
            mx, my = a[0] + b[0], a[1] + b[1]
            mL = math.hypot(mx, my)
            mx, my = mx / mL, my / mL
            c = mx * a[0] + my * a[1]
            nx, ny = mx / c, my / c
        left.append((x + nx * t / 2, y + ny * t / 2))
        right.append((x - nx * t / 2, y - ny * t / 2))
    return left + right[::-1]


# ---------------- housing ----------------
body = ybox(-BODY_W / 2, BODY_W / 2, Y_FRONT, Y_BACK, -BODY_H / 2, BODY_H / 2)
body = body.edges("|Y").fillet(BODY_R_CORNER)
body = body.faces("<Y").edges().fillet(BODY_R_EDGE)
body = body.faces(">Y").edges().fillet(BODY_R_EDGE)

# ---------------- boss + keys on the back ----------------
flange = ycyl(FLANGE_D, Y_BACK - 0.1, Y_BACK + FLANGE_T)
key_z0 = FLANGE_D / 2 - 0.8
key_z1 = BODY_H / 2 - KEY_TOP_GAP
for s in (1, -1):
    kb = ybox(-KEY_W / 2, KEY_W / 2, Y_BACK - 0.1, Y_BACK + FLANGE_T,
              min(s * key_z0, s * key_z1), max(s * key_z0, s * key_z1))
    flange = flange.union(kb)

# ---------------- bushing and shaft ----------------
y_b0 = Y_BACK + FLANGE_T
y_b1 = y_b0 + BUSH_L
y_s0 = y_b1 + NECK_L
y_s1 = y_s0 + SHAFT_L
bushing = ycyl(BUSH_D, y_b0 - 0.1, y_b1)
neck = ycyl(NECK_D, y_b1 - 0.1, y_s0 + 0.1)
shaft = ycyl(SHAFT_D, y_s0, y_s1)
shaft = shaft.faces(">Y").edges().fillet(SHAFT_END_R)
flat_cut = ybox(-SHAFT_D, SHAFT_D, y_s0 + FLAT_START, y_s1 + 1.0, FLAT_H, SHAFT_D)
shaft = shaft.cut(flat_cut)

part = body.union(flange).union(bushing).union(neck).union(shaft)

# ---------------- bent PCB pins ----------------
def pin(side, z):
    """side=-1 for -X pins, +1 for +X pins."""
    reach = PIN_OUT_L if side < 0 else PIN_OUT_R
    face_x = side * BODY_W / 2
    x_out = side * (BODY_W / 2 + reach)
    x_in = x_out - side * PIN_T
    y_back = Y_FRONT + PIN_Y_OFF
    y_front = y_back - PIN_T
    seg1 = ybox(min(face_x - side * 0.3, x_out), max(face_x - side * 0.3, x_out),
                y_front, y_back, z - PIN_W / 2, z + PIN_W / 2)
    seg2 = ybox(min(x_in, x_out), max(x_in, x_out),
                Y_FRONT - PIN_LEN, y_back, z - PIN_W / 2, z + PIN_W / 2)
    seg2 = seg2.faces("<Y").edges("|X").chamfer(PIN_CH)
    return seg1.union(seg2)


for z in (PIN_PITCH, 0.0, -PIN_PITCH):
    part = part.union(pin(-1, z))
for z in (PIN_PITCH, -PIN_PITCH):
    part = part.union(pin(1, z))

# ---------------- zig-zag mounting tabs (top and bottom) ----------------
# centre line in (Y relative to front face, Z relative to top face)
TAB_PROFILE = [(0.8, 0.04), (0.06, 0.3), (-0.4, -0.08), (-1.7, 0.36),
               (-TAB_REACH - 0.4, -0.12)]


def make_tab():
    pts = [(Y_FRONT + u, BODY_H / 2 + v) for (u, v) in TAB_PROFILE]
    outline = thick_polyline(pts, TAB_T)
    tab = (cq.Workplane("YZ", origin=(-TAB_W / 2, 0, 0))
           .polyline(outline).close().extrude(TAB_W))
    # rounded tip seen from above
    yc = Y_FRONT - TAB_REACH + TAB_W / 2
    stadium = (cq.Workplane("XY", origin=(0, 0, BODY_H / 2 - 2.0))
               .center(0, yc).circle(TAB_W / 2).extrude(4.0)
               .union(ybox(-TAB_W / 2, TAB_W / 2, yc, Y_FRONT + 2.0,
                           BODY_H / 2 - 2.0, BODY_H / 2 + 2.0)))
    return tab.intersect(stadium)


tab_top = make_tab()
tab_bot = make_tab().mirror("XY")
part = part.union(tab_top).union(tab_bot)

# ---------------- thin side tab at the back, -X side ----------------
side_tab = ybox(-BODY_W / 2 - SIDE_TAB_T, -BODY_W / 2 + 0.05,
                Y_BACK - SIDE_TAB_IN, Y_BACK + SIDE_TAB_OUT,
                -SIDE_TAB_H / 2, SIDE_TAB_H / 2)
side_tab = side_tab.edges("|Y").fillet(SIDE_TAB_T * 0.45)
part = part.union(side_tab)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
